import cadquery as cq

# Torus (solid ring / donut)
MINOR_R = 20.0    # tube (cross-section) radius
MAJOR_R = 28.5    # radius of the tube centre-line about the Z axis
SEAM_ANGLE = 135.0 # where the revolve seam meridian sits (deg about Z, from +X)

# Circular cross-section in the XZ plane; start the circle at the innermost
# point so the profile seam lies on the inside of the hole.
profile_edge = cq.Edge.makeCircle(
    MINOR_R, cq.Vector(MAJOR_R, 0, 0), cq.Vector(0, 1, 0), 270, 630
)
profile_face = cq.Face.makeFromWires(cq.Wire.assembleEdges([profile_edge]))

# Revolve the section a full turn about the vertical (Z) axis
ring = cq.Solid.revolve(profile_face, 360, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1))
ring = ring.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_ANGLE)

result = cq.Workplane("XY").add(ring)

VIEW = {"azimuth": 45, "elevation": 26}
